import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 297.0        # box length along X (tube open at both ends)
D = 64.0         # box depth along Y (front face at Y=0, back face at Y=D)
H = 135.0        # box height along Z
T = 3.3          # sheet thickness
R_BEND = 0.5     # inner bend radius of the tube corners

# top slots (45 deg slanted parallelograms with rounded corners)
N_SLOTS = 4
SLOT_PITCH = 69.5
SLOT_X0 = 1.5        # shift of the slot row towards +X
SLOT_Y0 = 0.6        # shift of the slot row towards the back
SLOT_W = 42.6        # width measured along X (outline)
SLOT_DY = 42.3       # extent along Y (outline)
SLOT_SLANT = 45.0    # slant of the long sides (deg from X)
SLOT_R_ACUTE = 4.0   # corner radius of the cut at the two 45 deg corners
SLOT_R_OBTUSE = 9.5  # corner radius of the cut at the two 135 deg corners
SLOT_RIM_R = 2.0     # rounding of the slot top edge

# diagonal internal partition (bottom of -X end up to top of +X end)
PLATE_T = 2.0

# wedge lip along the upper back face
LIP_TOP_DROP = 12.0   # lip top below box top
LIP_OUT = 22.0        # how far the lip sticks out behind the back face
LIP_H = 23.0          # lip height where it meets the back wall
LIP_END = 20.0        # lip ends (at the wall) measured from each box end
LIP_R = 3.0           # rounding of the lip nose

# triangular mounting ears at the bottom of the back face
EAR_BASE = 47.0       # ear base length along the wall
EAR_OUT = 24.0        # ear reach behind the back face
EAR_HOLE_D = 6.0
EAR_HOLE_Y = 10.0     # hole distance behind the back face

# small locating tab at the -X end of the floor
END_TAB_W = 16.0
END_TAB_L = 8.0

# ---------------- rectangular tube ----------------
ro = R_BEND + T
outer = (cq.Workplane("YZ").center(D / 2, H / 2).rect(D, H).extrude(L)
         .edges("|X").fillet(ro))
inner = (cq.Workplane("YZ").center(D / 2, H / 2).rect(D - 2 * T, H - 2 * T)
         .extrude(L).edges("|X").fillet(R_BEND))
body = outer.cut(inner)

# ---------------- diagonal partition plate ----------------
ang = math.degrees(math.atan2(H, L))
diag = math.hypot(L, H)
plate = (cq.Workplane("XY").box(diag * 1.2, D, PLATE_T)
         .rotate((0, 0, 0), (0, 1, 0), -ang)
         .translate((L / 2, D / 2, H / 2)))
# trim to the outer tube envelope so its edges run flush on the front/back faces
plate = plate.intersect(outer)

# ---------------- slots in the top ----------------
# the through-cut is shrunk by half the rim radius on every side, so the
# rounded rim straddles the nominal slot outline
cut_dy = SLOT_DY - SLOT_RIM_R
cut_w = SLOT_W - SLOT_RIM_R / math.sin(math.radians(SLOT_SLANT))
dx_slant = cut_dy / math.tan(math.radians(SLOT_SLANT))
x_first = L / 2 + SLOT_X0 - SLOT_PITCH * (N_SLOTS - 1) / 2
for i in range(N_SLOTS):
    cx = x_first + i * SLOT_PITCH
    cy = D / 2 + SLOT_Y0
    pts = [
        (cx - cut_w / 2 - dx_slant / 2, cy - cut_dy / 2),
        (cx + cut_w / 2 - dx_slant / 2, cy - cut_dy / 2),
        (cx + cut_w / 2 + dx_slant / 2, cy + cut_dy / 2),
        (cx - cut_w / 2 + dx_slant / 2, cy + cut_dy / 2),
    ]
    cutter = cq.Workplane("XY").polyline(pts).close().extrude(T + 2.0)
    for k, (px, py) in enumerate(pts):
        r = SLOT_R_ACUTE if k in (0, 2) else SLOT_R_OBTUSE
        cutter = cutter.edges(cq.selectors.BoxSelector(
            (px - 0.5, py - 0.5, -1.0), (px + 0.5, py + 0.5, T * 5))).fillet(r)
    cutter = cutter.translate((0, 0, H - T - 1.0))
    body = body.cut(cutter)
    # rounded (formed) rim along the top edge of every slot
    bx0 = min(p[0] for p in pts) - 1.0
    bx1 = max(p[0] for p in pts) + 1.0
    body = body.edges(cq.selectors.BoxSelector(
        (bx0, cy - SLOT_DY / 2 - 1.0, H - 0.2),
        (bx1, cy + SLOT_DY / 2 + 1.0, H + 0.2))).fillet(SLOT_RIM_R)

# ---------------- wedge lip on the back face ----------------
z_top = H - LIP_TOP_DROP
lip = (cq.Workplane("YZ")
       .polyline([(D - T, z_top), (D + LIP_OUT, z_top),
                  (D, z_top - LIP_H), (D - T, z_top - LIP_H)]).close()
       .extrude(L))
lip = lip.edges("|X").edges(">Y").fillet(LIP_R)
# 45 deg mitred ends in plan (parallel to the mounting ears)
span = LIP_OUT + 5.0
plan = (cq.Workplane("XY").workplane(offset=z_top - LIP_H - 1)
        .polyline([(LIP_END - T, D - T), (L - LIP_END + T, D - T),
                   (L - LIP_END - span, D + span), (LIP_END + span, D + span)])
        .close().extrude(LIP_H + 2))
lip = lip.intersect(plan)
body = body.union(lip)


# ---------------- triangular mounting ears ----------------
def ear(x0, sgn):
    pts = [(x0, D - T), (x0, D), (x0 + sgn * EAR_OUT, D + EAR_OUT),
           (x0 + sgn * EAR_BASE, D), (x0 + sgn * EAR_BASE, D - T)]
    e = cq.Workplane("XY").polyline(pts).close().extrude(T)
    e = e.edges("|Z").edges(">Y").fillet(3.0)
    hole = (cq.Workplane("XY").center(x0 + sgn * EAR_BASE / 2, D + EAR_HOLE_Y)
            .circle(EAR_HOLE_D / 2).extrude(T))
    return e.cut(hole)

body = body.union(ear(0.0, 1)).union(ear(L, -1))

# ---------------- small tab at the -X end of the floor ----------------
tab = (cq.Workplane("XY").center(-END_TAB_L / 2 + T, D / 2)
       .rect(END_TAB_L + 2 * T, END_TAB_W).extrude(T))
tab = tab.edges("|Y").edges("<X").fillet(T * 0.45)   # rounded tab nose
body = body.union(tab)

body = body.union(plate, clean=False)

result = body
